"""Hinged cover plate: filleted top plate with four tapped holes, a shallow
perimeter rim underneath (open pocket inside), and a hinge tab with pin
holes along the -X end."""
import cadquery as cq

# ---- driving dimensions (mm) ----
L = 150.0          # plate length (X)
W = 99.0           # plate width (Y)
T1 = 6.5           # top plate thickness
T2 = 3.3           # depth of the perimeter rim under the plate
STEP_IN = 3.3      # inset of the rim on +X, +Y, -Y sides (flush at -X)
RIM_W = 3.0        # rim wall width
R_TOP = 1.5        # fillet on the top edges
R_BOT = 0.5        # small round on the plate's lower outer edges
R_CORNER = 1.8     # vertical corner radius on the +X corners

TAB_T = 6.5        # hinge tab thickness (X)
TAB_IN = 6.5       # tab inset from the Y sides
TAB_H = 12.5       # tab height below the rim
PIN_D = 4.0        # pin holes in both tab ends (along Y)
PIN_DEPTH = 8.0
PIN_Z = 4.5        # pin hole centre below the rim

HOLE_D = 12.5      # tapped holes (threads left out)
HOLE_DX = 48.7     # hole spacing in X
HOLE_DY = 30.0     # hole spacing in Y
HOLE_OY = -2.5     # hole pattern offset in Y

# ---- top plate ----
top = cq.Workplane("XY").box(L, W, T1, centered=(True, True, False))
top = top.edges("|Z and >X").fillet(R_CORNER)
top = top.faces(">Z").edges().fillet(R_TOP)
top = top.faces("<Z").edges("not <X").fillet(R_BOT)

# ---- perimeter rim under the plate (flush with the -X end) ----
rim_len = L - STEP_IN
rim_wid = W - 2 * STEP_IN
rim_outer = (cq.Workplane("XY")
             .box(rim_len, rim_wid, T2, centered=(False, True, False))
             .translate((-L / 2, 0, -T2)))
rim_inner = (cq.Workplane("XY")
             .box(rim_len - 2 * RIM_W, rim_wid - 2 * RIM_W, T2 + 2,
                  centered=(False, True, False))
             .translate((-L / 2 + RIM_W, 0, -T2 - 1)))
rim = rim_outer.cut(rim_inner)

# ---- hinge tab at the -X end ----
tab_len = W - 2 * TAB_IN
tab = (cq.Workplane("XY")
       .box(TAB_T, tab_len, TAB_H + T2, centered=(False, True, False))
       .translate((-L / 2, 0, -T2 - TAB_H)))
pin_x = -L / 2 + TAB_T / 2
pin_z = -T2 - PIN_Z
for sgn in (-1, 1):
    pin = (cq.Workplane("XZ", origin=(0, sgn * tab_len / 2, 0))
           .center(pin_x, pin_z).circle(PIN_D / 2)
           .extrude(PIN_DEPTH if sgn > 0 else -PIN_DEPTH))
    tab = tab.cut(pin)

body = top.union(rim).union(tab)

# ---- tapped holes ----
pts = [(sx * HOLE_DX / 2, HOLE_OY + sy * HOLE_DY / 2)
       for sx in (-1, 1) for sy in (-1, 1)]
cutter = (cq.Workplane("XY").workplane(offset=-1)
          .pushPoints(pts).circle(HOLE_D / 2).extrude(T1 + 2))
result = body.cut(cutter)

VIEW = {"azimuth": 45, "elevation": 26}
